"""Hex-bodied holder with a thin-walled tube.

Hex prism (flats facing +/-X, corners pointing +/-Y) with filleted vertical and top
edges; a tube rises from the centre of the top face through an elliptical foot blend.
The tube carries a stepped internal bore (round -> double-D -> small drilled hole),
a flat-bottomed side window near its tip and a narrow slit down its -X side.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HEX_AF = 21.8          # hex across flats (flats face +/-X, corners point +/-Y)
HEX_H = 48.0           # hex body height
HEX_TOP_R = 0.6        # fillet on the top hex edges (bottom edges stay sharp)
HEX_VERT_R = 0.85      # fillet on the six vertical hex edges

TUBE_OD = 5.0          # tube outer diameter
TUBE_L = 48.4          # tube length above the hex top face
BLEND_W = 2.7          # radial extent of the elliptical blend at the tube foot
BLEND_H = 4.0          # height of that blend up the tube

BORE_D = 4.05          # main bore diameter (from the tip)
BORE_DEPTH = 30.0      # depth of the full-round bore
FLAT_HALF = 1.10       # half width of the double-D section below the bore
FLAT_DEPTH = 10.0      # length of the double-D section
PIN_D = 1.55           # small central hole at the bottom
PIN_DEPTH = 6.0        # cylindrical depth of that hole
PIN_TIP_ANGLE = 90.0   # included angle of the conical hole bottom

# side window near the tip, on the -X side (flat-bottomed cross cut)
WIN_TOP = 5.0          # distance from tube tip to top of window
WIN_H = 2.6            # window height
WIN_X = -1.25          # material removed where x < WIN_X

# narrow slit running down the -X side from the window toward the base
SLIT_W = 0.48          # slit width
SLIT_R_IN = 1.53       # slit cuts radially inward to this radius (round end)
SLIT_BOTTOM = 5.4      # slit ends this far above the hex top face

# ---------------- hex body ----------------
R_corner = HEX_AF / 2.0 / math.cos(math.radians(30))
hex_pts = [
    (R_corner * math.cos(math.radians(90 + 60 * i)),
     R_corner * math.sin(math.radians(90 + 60 * i)))
    for i in range(6)
]
body = cq.Workplane("XY").polyline(hex_pts).close().extrude(HEX_H)
body = body.edges("|Z").fillet(HEX_VERT_R)
body = body.faces(">Z").edges().fillet(HEX_TOP_R)

# ---------------- tube with elliptical foot blend (revolved profile) ----------------
Z_TIP = HEX_H + TUBE_L
R_T = TUBE_OD / 2.0
tube_profile = (
    cq.Workplane("XZ")
    .moveTo(0, Z_TIP)
    .lineTo(R_T, Z_TIP)
    .lineTo(R_T, HEX_H + BLEND_H)
    # quarter ellipse, concave, tangent to the tube wall and to the hex top face
    .ellipseArc(BLEND_W, BLEND_H, angle1=180, angle2=270, sense=1, startAtCurrent=True)
    .lineTo(R_T + BLEND_W, HEX_H - 1.0)     # small plug sunk into the hex body
    .lineTo(0, HEX_H - 1.0)
    .close()
)
tube = (
    tube_profile.revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), 180)      # put the surface seams on the -X side
)
part = body.union(tube)

# ---------------- internal bore: round -> double-D -> small drilled hole ----------------
z_ledge = Z_TIP - BORE_DEPTH
z_dd_bot = z_ledge - FLAT_DEPTH
z_pin_bot = z_dd_bot - PIN_DEPTH

bore = (
    cq.Workplane("XY", origin=(0, 0, z_ledge))
    .circle(BORE_D / 2.0)
    .extrude(BORE_DEPTH + 1.0)
)
r_b = BORE_D / 2.0
y_c = math.sqrt(r_b ** 2 - FLAT_HALF ** 2)
dd = (
    cq.Workplane("XY", origin=(0, 0, z_dd_bot))
    .moveTo(FLAT_HALF, -y_c)
    .lineTo(FLAT_HALF, y_c)
    .threePointArc((0, r_b), (-FLAT_HALF, y_c))
    .lineTo(-FLAT_HALF, -y_c)
    .threePointArc((0, -r_b), (FLAT_HALF, -y_c))
    .close()
    .extrude(FLAT_DEPTH)   # top face coincides with the bore bottom
)
tip_h = (PIN_D / 2.0) / math.tan(math.radians(PIN_TIP_ANGLE / 2.0))
pin_cyl = cq.Solid.makeCylinder(
    PIN_D / 2.0, PIN_DEPTH + 0.01, cq.Vector(0, 0, z_pin_bot), cq.Vector(0, 0, 1)
)
pin_tip = cq.Solid.makeCone(
    0.0, PIN_D / 2.0, tip_h, cq.Vector(0, 0, z_pin_bot - tip_h), cq.Vector(0, 0, 1)
)
pin = cq.Workplane("XY").add(pin_cyl.fuse(pin_tip).clean())
part = part.cut(bore).cut(dd).cut(pin)

# ---------------- side window near the tip (-X side) ----------------
win_z0 = Z_TIP - WIN_TOP - WIN_H
window = (
    cq.Workplane("XY")
    .box(TUBE_OD, TUBE_OD * 2, WIN_H, centered=(False, True, False))
    .translate((WIN_X - TUBE_OD, 0, win_z0))
)
part = part.cut(window)

# ---------------- narrow slit down the -X side ----------------
slit_top = win_z0 + 0.2
slit_bot = HEX_H + SLIT_BOTTOM
slit_len = slit_top - slit_bot
x_end = -SLIT_R_IN - SLIT_W / 2.0          # centre of the round slit end
slit = (
    cq.Workplane("XY", origin=(x_end - TUBE_OD, -SLIT_W / 2.0, slit_bot))
    .rect(TUBE_OD, SLIT_W, centered=False)
    .extrude(slit_len)
    .union(
        cq.Workplane("XY", origin=(x_end, 0, slit_bot))
        .circle(SLIT_W / 2.0)
        .extrude(slit_len)
    )
)
part = part.cut(slit)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
